"""Shallow circular housing / cover (cup) with a back plate.

Axis of revolution = X.  The back plate lies at x = 0 .. FLOOR, the open
side (front rim) faces +X.  The back plate carries a centre bore with a
4-hole bolt pattern, two lower mounting holes and a rectangular window with
rounded lower corners.  Back outer edge chamfered, floor/wall junction and
inner rim edge chamfered.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OD = 200.0          # outer diameter
H = 23.3            # overall depth (along X, open side toward +X)
WALL = 4.7          # side wall thickness
FLOOR = 6.2         # back plate (floor) thickness
BACK_CH = 3.0       # chamfer on the back outer edge
BASE_CH = 2.3       # chamfer between floor and inner wall
RIM_CH = 1.75       # chamfer on the inner edge of the front rim

CENTER_D = 18.5     # centre bore
BOLT_R = 17.5       # radius of the 4-hole pattern
BOLT_D = 5.8        # 4-hole pattern hole diameter
BOLT_N = 4
MOUNT_Y = 61.3      # lower mounting holes at (+-MOUNT_Y, MOUNT_Z)
MOUNT_Z = -61.0
MOUNT_D = 6.0

WIN_W = 107.5       # window cut-out width (along Y)
WIN_TOP = -43.5     # z of the window's top edge
WIN_BOT = -78.7     # z of the window's bottom edge
WIN_R = 11.0        # radius of the window's lower corners

R = OD / 2.0
RI = R - WALL

# seam placement (cosmetic only: keeps circle seams on hidden sides)
SEAM_OUT = math.radians(-50.0)
SEAM_IN = math.radians(180.0)


def yz_plane(x0, ang):
    """YZ workplane at x = x0 (normal +X) whose local x axis points at angle
    ang measured in the YZ plane from +Y toward +Z."""
    return cq.Workplane(
        cq.Plane(origin=(x0, 0, 0),
                 xDir=(0, math.cos(ang), math.sin(ang)),
                 normal=(1, 0, 0))
    )


def yz_pt(y, z, ang):
    """world (y, z) -> local 2D coords on yz_plane(., ang)"""
    c, s = math.cos(ang), math.sin(ang)
    return (y * c + z * s, -y * s + z * c)


def circle_edge(shape, x0, r0, tol=1e-3):
    """the circular edge of `shape` lying at x = x0 with radius r0"""
    for e in shape.Edges():
        if (e.geomType() == "CIRCLE" and abs(e.Center().x - x0) < tol
                and abs(e.radius() - r0) < tol):
            return e
    raise ValueError("edge not found")


# ---------------- main body ----------------
body = yz_plane(0, SEAM_OUT).circle(R).extrude(H)
body = body.faces("<X").edges().chamfer(BACK_CH)          # back outer edge

# cavity, open toward +X
cavity = yz_plane(FLOOR, SEAM_IN).circle(RI).extrude(H)
body = body.cut(cavity)

# chamfers: floor / inner-wall junction and inner edge of the front rim
solid = body.val()
solid = solid.chamfer(BASE_CH, None, [circle_edge(solid, FLOOR, RI)])
solid = solid.chamfer(RIM_CH, None, [circle_edge(solid, H, RI)])
body = cq.Workplane("XY").add(solid)

# ---------------- holes through the back plate ----------------
L = 3 * H
hp = yz_plane(-H, SEAM_IN)

centre = hp.circle(CENTER_D / 2).extrude(L)
bolt_pts = [
    (BOLT_R * math.cos(2 * math.pi * i / BOLT_N),
     BOLT_R * math.sin(2 * math.pi * i / BOLT_N))
    for i in range(BOLT_N)
]  # polar pattern (points only, so every hole keeps the same seam side)
bolts = hp.pushPoints(bolt_pts).circle(BOLT_D / 2).extrude(L)
mounts = (
    hp.pushPoints([yz_pt(MOUNT_Y, MOUNT_Z, SEAM_IN),
                   yz_pt(-MOUNT_Y, MOUNT_Z, SEAM_IN)])
    .circle(MOUNT_D / 2).extrude(L)
)

# window: rectangle with rounded lower corners, through the back plate
win_h = WIN_TOP - WIN_BOT
win = (
    cq.Workplane("YZ", origin=(-1.0, 0, 0))
    .center(0, (WIN_TOP + WIN_BOT) / 2)
    .rect(WIN_W, win_h)
    .extrude(FLOOR + 2.0)
)
win = win.edges("|X").edges("<Z").fillet(WIN_R)

result = body.cut(centre).cut(bolts).cut(mounts).cut(win)

VIEW = {"azimuth": 45, "elevation": 26}
